import math
import cadquery as cq

# ---------------------------------------------------------------------------
# Latch lever plate: flat front face (Y=0), features stepping toward +Y.
# X to the right, Z up.  All dimensions in millimetres.
# ---------------------------------------------------------------------------

# thicknesses (Y)
T_FULL = 6.3       # full body thickness
T_PLATE = 1.25     # thin front web
T_STEM = 2.9       # lower stem / hook tabs thickness

# left arm
ARM_X0, ARM_X1 = 0.0, 66.4
ARM_Z0, ARM_Z1 = 86.5, 110.3
STEP_W, STEP_Z = 5.1, 105.0      # small step at the top-left end
STEP_R = 5.0                     # rounded corner above the step

# stem
STEM_X0, STEM_X1 = 66.4, 77.4
STEM_W = STEM_X1 - STEM_X0
STEM_XC = 0.5 * (STEM_X0 + STEM_X1)

# right arm block
RARM_X1 = 105.0
RARM_Z0, RARM_Z1 = ARM_Z1, 135.1

# ear (tilted tab carrying a nut trap)
EAR_C = (66.7, 137.1)
EAR_ANG = 124.4         # axis direction, degrees from +X
EAR_W = 8.4
EAR_END = 5.0           # end of the tab beyond the hole centre
EAR_R = 3.0

# lower boss (nut trap) left of the stem
BOSS_X0, BOSS_Z1 = 58.3, 119.1  # left edge / top of the boss
BOSS_R = 2.0                    # rounded top-left corner
BOSS_HEX = (62.3, 114.5)        # nut trap centre (hex turned 30 deg)

# hexagonal nut traps (through the ear and the lower boss)
HEX_AF = 5.4

# hook tabs under the left arm
TAB_W = 4.4
TAB_FOOT = 3.5
TAB_FOOT_H = 3.5
TAB_Z0 = 77.0
TAB_XS = (22.6, STEM_X0)   # right edges of the two tab posts

# back-side bands (Z)
TOPBAND_Z0 = 102.9
RAIL_Z0, RAIL_Z1 = ARM_Z0, 91.2

# gaps in the top band (X ranges) -> thin web only
GAPS = [(26.9, 35.8), (46.9, BOSS_X0)]
LEDGE_H, LEDGE_D = 2.9, 2.0      # stepped-back foot under the middle block
BOSS_STEP_D = 1.0                # shallow step under the lower boss
HEAD_RECESS_X1 = 76.9            # recess in the back of the stem head
HEAD_RECESS_Z1 = 109.7
HEAD_RECESS_R = 2.5
HEAD_RECESS_D = 2.0
HOOK_W = 1.5                     # width of the hook rib
HOOK_BLOCK_X = (17.2, 26.9)

# pin at the bottom of the stem
PIN_D = 8.4
PIN_Y1 = 11.4
PIN_FILLET = 0.4

# vertical grooves in the back of the right arm block
GROOVE_X = (79.4, 94.5)
GROOVE_R = 1.6
GROOVE_L = 4.0                   # grooves only notch the top edge
CHAN_W = 7.2                     # shallow ramped channels below the grooves
CHAN_D = 1.4
CHAN_Z0 = 113.9
STOP_W, STOP_H = 3.6, 2.6        # small stops at the channel bottoms

SMALL_HOLE_D = 2.0
RAIL_HOLE_D = 2.4
SMALL_HOLE_DEPTH = 2.5


def prism(sketch_wp, y0, y1):
    """extrude an XZ-workplane sketch from Y=y0 to Y=y1"""
    return sketch_wp.extrude(-(y1 - y0)).translate((0, y0, 0))


def xz():
    return cq.Workplane("XZ")


def box(x0, x1, z0, z1, y0, y1):
    return cq.Workplane("XY").box(x1 - x0, y1 - y0, z1 - z0, centered=False).translate((x0, y0, z0))


# ---------------- outline pieces (full thickness) ----------------
def body_outline(y0, y1):
    parts = []
    # left arm with the step + rounded corner
    cx, cz = STEP_W + STEP_R, ARM_Z1 - STEP_R
    arm = (xz().moveTo(ARM_X0, ARM_Z0)
           .lineTo(ARM_X1 + 0.5, ARM_Z0)
           .lineTo(ARM_X1 + 0.5, ARM_Z1)
           .lineTo(cx, ARM_Z1)
           .threePointArc((cx - STEP_R * math.cos(math.pi / 4), cz + STEP_R * math.sin(math.pi / 4)),
                          (STEP_W, cz))
           .lineTo(STEP_W, STEP_Z)
           .lineTo(ARM_X0, STEP_Z)
           .close())
    parts.append(prism(arm, y0, y1))
    # stem with round bottom, up to the right arm top
    stem = (xz().moveTo(STEM_X0, STEM_W / 2)
            .threePointArc((STEM_XC, 0.0), (STEM_X1, STEM_W / 2))
            .lineTo(STEM_X1, RARM_Z1)
            .lineTo(STEM_X0, RARM_Z1)
            .close())
    parts.append(prism(stem, y0, y1))
    # right arm
    parts.append(box(STEM_X1 - 0.5, RARM_X1, RARM_Z0, RARM_Z1, y0, y1))
    # ear: tilted rounded tab
    a = math.radians(EAR_ANG)
    ux, uz = math.cos(a), math.sin(a)
    nx, nz = -uz, ux
    L_in = 22.0             # how far the tab runs back into the body
    cxe, cze = EAR_C
    # local rectangle u in [-L_in, EAR_END], v in [-W/2, W/2], outer corners rounded
    r = EAR_R
    hw = EAR_W / 2

    def P(u, v):
        return (cxe + u * ux + v * nx, cze + u * uz + v * nz)

    ear = (xz().moveTo(*P(-L_in, -hw))
           .lineTo(*P(EAR_END - r, -hw))
           .threePointArc(P(EAR_END - r + r * math.cos(math.pi / 4), -hw + r - r * math.sin(math.pi / 4)),
                          P(EAR_END, -hw + r))
           .lineTo(*P(EAR_END, hw - r))
           .threePointArc(P(EAR_END - r + r * math.cos(math.pi / 4), hw - r + r * math.sin(math.pi / 4)),
                          P(EAR_END - r, hw))
           .lineTo(*P(-L_in, hw))
           .close())
    parts.append(prism(ear, y0, y1))
    # lower boss with rounded top-left corner
    bcx, bcz = BOSS_X0 + BOSS_R, BOSS_Z1 - BOSS_R
    boss = (xz().moveTo(BOSS_X0, ARM_Z1 - 0.5)
            .lineTo(STEM_X0 + 0.5, ARM_Z1 - 0.5)
            .lineTo(STEM_X0 + 0.5, BOSS_Z1)
            .lineTo(bcx, BOSS_Z1)
            .threePointArc((bcx - BOSS_R * math.cos(math.pi / 4), bcz + BOSS_R * math.sin(math.pi / 4)),
                           (BOSS_X0, bcz))
            .close())
    parts.append(prism(boss, y0, y1))
    # hook tabs
    for xr in TAB_XS:
        xl = xr - TAB_W
        tab = (xz().moveTo(xr + 0.5, ARM_Z0 + 0.5)
               .lineTo(xl, ARM_Z0 + 0.5)
               .lineTo(xl, TAB_Z0 + TAB_FOOT_H)
               .lineTo(xl - TAB_FOOT, TAB_Z0 + TAB_FOOT_H)
               .lineTo(xl - TAB_FOOT, TAB_Z0)
               .lineTo(xr + 0.5, TAB_Z0)
               .close())
        parts.append(prism(tab, y0, y1))
    out = parts[0]
    for p in parts[1:]:
        out = out.union(p)
    return out


body = body_outline(0.0, T_FULL)

# ---------------- back-side relief ----------------
cuts = []
# thin web band across the left arm and stem
cuts.append(box(-1, STEM_X1 + 1, RAIL_Z1, TOPBAND_Z0, T_PLATE, T_FULL + 1))
# lower stem and tabs are thinner
cuts.append(box(-1, STEM_X1 + 1, -1, RAIL_Z0, T_STEM, T_FULL + 1))
# gaps in the top band
for gx0, gx1 in GAPS:
    cuts.append(box(gx0, gx1, TOPBAND_Z0 - 0.01, ARM_Z1 + 1, T_PLATE, T_FULL + 1))
# pocket inside the hook rib
hx0 = STEP_W + HOOK_W
hx1 = HOOK_BLOCK_X[0]
hz1 = ARM_Z1 - HOOK_W
hr = STEP_R - HOOK_W
hcx, hcz = STEP_W + STEP_R, ARM_Z1 - STEP_R
hook_pocket = (xz().moveTo(hx0, TOPBAND_Z0 - 0.01)
               .lineTo(hx1, TOPBAND_Z0 - 0.01)
               .lineTo(hx1, hz1)
               .lineTo(hcx, hz1)
               .threePointArc((hcx - hr * math.cos(math.pi / 4), hcz + hr * math.sin(math.pi / 4)), (hx0, hcz))
               .close())
cuts.append(prism(hook_pocket, T_PLATE, T_FULL + 1))

# stepped-back lower edge of the middle block
cuts.append(box(GAPS[0][1] - 0.01, GAPS[1][0] + 0.01, TOPBAND_Z0 - 0.01, TOPBAND_Z0 + LEDGE_H,
                T_FULL - LEDGE_D, T_FULL + 1))
# shallow step under the lower boss
cuts.append(box(BOSS_X0 - 0.01, STEM_X0, TOPBAND_Z0 - 0.01, HEAD_RECESS_Z1 + 0.2,
                T_FULL - BOSS_STEP_D, T_FULL + 1))
# recess in the back of the stem head with a rounded upper corner
rx0, rx1 = STEM_X0, HEAD_RECESS_X1
rz1, rr = HEAD_RECESS_Z1, HEAD_RECESS_R
head_recess = (xz().moveTo(rx0, TOPBAND_Z0 - 0.01)
               .lineTo(rx1, TOPBAND_Z0 - 0.01)
               .lineTo(rx1, rz1)
               .lineTo(rx0 + rr, rz1)
               .threePointArc((rx0 + rr - rr * math.cos(math.pi / 4), rz1 - rr + rr * math.sin(math.pi / 4)),
                              (rx0, rz1 - rr))
               .close())
cuts.append(prism(head_recess, T_FULL - HEAD_RECESS_D, T_FULL + 1))

for c in cuts:
    body = body.cut(c)

# ---------------- hexagonal nut traps (through) ----------------
def hex_hole(cx, cz, rot):
    hp = xz().center(cx, cz).transformed(rotate=(0, 0, rot)).polygon(6, HEX_AF / math.cos(math.pi / 6))
    return prism(hp, -1.0, T_FULL + 1)


body = body.cut(hex_hole(EAR_C[0], EAR_C[1], 0.0))
body = body.cut(hex_hole(BOSS_HEX[0], BOSS_HEX[1], 30.0))

# ---------------- ramped channels + grooves in the back of the right arm ----------------
for gx in GROOVE_X:
    # channel floor ramps from flush at the top edge down to CHAN_D deep
    ramp = (cq.Workplane("YZ").moveTo(T_FULL - CHAN_D, CHAN_Z0)
            .lineTo(T_FULL + 1, CHAN_Z0)
            .lineTo(T_FULL + 1, RARM_Z1 + 1)
            .lineTo(T_FULL, RARM_Z1 + 1)
            .lineTo(T_FULL, RARM_Z1)
            .close()
            .extrude(CHAN_W)
            .translate((gx - CHAN_W / 2, 0, 0)))
    body = body.cut(ramp)
    g = cq.Workplane("XY").cylinder(GROOVE_L + 1, GROOVE_R, centered=(True, True, False)) \
        .translate((gx, T_FULL, RARM_Z1 - GROOVE_L))
    body = body.cut(g)
    stop = box(gx - STOP_W / 2, gx + STOP_W / 2, CHAN_Z0 - 0.01, CHAN_Z0 + STOP_H,
               T_FULL - CHAN_D - 0.2, T_FULL - 0.2)
    body = body.union(stop)

# ---------------- small blind holes on the back ----------------
small_holes = [
    (73.5, 88.9, RAIL_HOLE_D), (41.5, 88.9, RAIL_HOLE_D), (5.5, 88.9, RAIL_HOLE_D),   # rail
    (21.9, 108.0, SMALL_HOLE_D),                  # hook block
    (102.0, 123.0, SMALL_HOLE_D), (71.0, 122.0, SMALL_HOLE_D),   # right arm block / stem head
]
for hx, hz, hd in small_holes:
    h = prism(xz().center(hx, hz).circle(hd / 2), T_FULL - SMALL_HOLE_DEPTH, T_FULL + 1)
    body = body.cut(h)
# small hole in the stepped face under the lower boss
body = body.cut(prism(xz().center(62.4, 105.5).circle(SMALL_HOLE_D / 2),
                      T_FULL - BOSS_STEP_D - SMALL_HOLE_DEPTH, T_FULL))

# ---------------- pin at the stem foot ----------------
pin = prism(xz().center(STEM_XC, STEM_W / 2).transformed(rotate=(0, 0, -90)).circle(PIN_D / 2),
            T_STEM - 0.01, PIN_Y1)
pin = pin.faces(">Y").edges().fillet(PIN_FILLET)
body = body.union(pin)

result = body
